import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm).  X = width, Y = depth (front is -Y), Z = height.
# ---------------------------------------------------------------------------
XL, XR = -69.75, 69.75          # overall width of the top frame
H_TOP = 236.5                   # top of the frame

# main (front) block
BX0, BX1 = 3.5, 69.75           # upper block X range
LX0 = -8.35                     # left edge of lower section
YF = -25.5                      # front face
YB = -6.2                       # back face of front block
YBK = 21.9                      # back face of lower wedge
Z_BLK_TOP = 161.8               # top of block at the front (= frame bottom)
Z_SLOPE = 72.0                  # front face starts sloping back here
BEND = 8.0                      # length of the soft bend front->slope
Y_SLOPE_BOT = 20.9              # slope meets the bottom here
Z_WEDGE_TOP = 47.0              # top of lower solid wedge
K_SLOPE = (Y_SLOPE_BOT - YF) / Z_SLOPE
WALL = 3.0                      # shell wall of the ribbed block
RIB = 2.5                       # internal rib thickness

# side arm
ARM_X0 = -45.95                 # arm tip
ARM_ZT, ARM_ZB = 117.0, 104.3   # arm top / bottom at the front face
ARM_K = 0.548                   # dZ/dY fall of the arm faces toward the back
ARM_YC = 18.5                   # where the arm's truss ends on the left wall

# top frame (wedge of two X-braced plates)
FR_T = 3.0                      # plate thickness
FR_YB = 11.4                    # back face of the frame
FR_Y0 = -5.6                    # front line Y at Z_BLK_TOP
FR_K = 0.2151                   # dY/dZ of tilted front plate
FR_ZC = 170.5                   # lower edge of the front X plate

# holes / bolts
BIG_HOLE_D = 26.5
BIG_HOLE_X = (12.05, 48.75)
BIG_HOLE_Z = 22.8
HEAD_D, HEAD_L = 9.0, 5.0
SHAFT_D, SHAFT_L = 4.2, 4.0


def prism_yz(pts, x0, x1):
    """Polygon in (Y,Z) extruded along +X from x0 to x1."""
    return (cq.Workplane("YZ", origin=(x0, 0, 0))
            .polyline(pts).close().extrude(x1 - x0))


def prism_xz(pts, y0, y1):
    """Polygon in (X,Z) extruded along Y from y0 to y1."""
    return (cq.Workplane("XZ", origin=(0, y1, 0))
            .polyline(pts).close().extrude(y1 - y0))


def prism_xy(pts, z0, z1):
    return (cq.Workplane("XY", origin=(0, 0, z0))
            .polyline(pts).close().extrude(z1 - z0))


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl_solid(p, d, dia, length):
    return cq.Solid.makeCylinder(dia / 2.0, length, cq.Vector(*p),
                                 cq.Vector(*d).normalized())


def bolt_solids(p, d, head_d=HEAD_D, head_l=HEAD_L, shaft_d=SHAFT_D,
                shaft_l=SHAFT_L):
    p = cq.Vector(*p)
    d = cq.Vector(*d).normalized()
    head = cq.Solid.makeCylinder(head_d / 2.0, head_l + 0.6, p - d * 0.6, d)
    shaft = cq.Solid.makeCylinder(shaft_d / 2.0, shaft_l + 0.5,
                                  p + d * (head_l - 0.5), d)
    return [head, shaft]


def group(solids):
    wp = cq.Workplane("XY")
    for s in solids:
        wp = wp.add(s.val() if isinstance(s, cq.Workplane) else s)
    return wp


def y_slope(z):
    return YF + (Z_SLOPE - z) * K_SLOPE


def frame_y(z):
    return FR_Y0 + (z - Z_BLK_TOP) * FR_K


def arm_z(y, z_front):
    return z_front - (y - YF) * ARM_K


# ---------------------------------------------------------------------------
# Main block (front plate body, sloped lower part, back wedge, left wall)
# ---------------------------------------------------------------------------
blk_xz = prism_xz([(LX0, -1.0), (BX1, -1.0), (BX1, 180), (BX0, 180),
                   (BX0, ARM_ZT), (ARM_X0, ARM_ZT), (ARM_X0, ARM_ZB),
                   (LX0, ARM_ZB)], YF - 1.0, YBK + 1.0)
# side profile: the front is one smooth spline face - vertical, a soft bend,
# then the straight slope down to the back bottom edge
_th = math.atan(K_SLOPE)                      # slope angle from vertical
_d = (math.sin(_th), -math.cos(_th))
_front = [(YF, Z_BLK_TOP), (YF, Z_SLOPE + BEND),
          (YF + BEND * _d[0], Z_SLOPE + BEND * _d[1]), (Y_SLOPE_BOT, 0.0)]
blk_yz = (cq.Workplane("YZ", origin=(ARM_X0 - 1, 0, 0))
          .moveTo(*_front[0])
          .spline(_front[1:], tangents=[(0, -1), (0, -1), _d, _d], includeCurrent=True)
          .lineTo(YBK, 0.0).lineTo(YBK, Z_WEDGE_TOP).lineTo(YB, Z_WEDGE_TOP)
          .lineTo(YB, Z_BLK_TOP).lineTo(3.0, Z_BLK_TOP).lineTo(frame_y(FR_ZC), FR_ZC)
          .close().extrude(BX1 - ARM_X0 + 2))
block = blk_xz.intersect(blk_yz)
# the arm's top falls toward the back
block = block.cut(prism_yz([(YF - 2, arm_z(YF - 2, ARM_ZT)), (YB + 2, arm_z(YB + 2, ARM_ZT)),
                            (YB + 2, 125.0), (YF - 2, 125.0)], ARM_X0 - 1, BX0))

lwall = prism_yz([(YB - 0.5, Z_WEDGE_TOP - 0.5), (YBK, Z_WEDGE_TOP - 0.5),
                  (YBK, arm_z(YBK, ARM_ZT)), (YB - 0.5, arm_z(YB - 0.5, ARM_ZT))],
                 LX0, BX0)

# side arm: a slab between two parallel planes falling toward the back,
# clipped in plan by an oblique back edge that runs onto the left wall
arm_band = prism_yz([(YF + 0.5, arm_z(YF + 0.5, ARM_ZT)), (YF + 0.5, arm_z(YF + 0.5, ARM_ZB)),
                     (YBK, arm_z(YBK, ARM_ZB)), (YBK, arm_z(YBK, ARM_ZT))],
                    ARM_X0, BX0 + 0.5)
arm_plan = prism_xy([(ARM_X0, YF - 1), (BX0, YF - 1), (BX0, ARM_YC),
                     (LX0, ARM_YC), (ARM_X0, YB)], 60, 130)
arm = arm_band.intersect(arm_plan)

block = block.union(group([lwall, arm]))

# --- cutters -----------------------------------------------------------------
cutters = []
# window through the left wall
cutters.append(prism_yz([(-2.9, 86.5), (18.4, 75.0), (18.4, 49.6), (-2.9, 49.6)],
                        LX0 - 2, BX0 + 2).edges("|X").fillet(3.0))
# waffle pockets in the back of the front block
POCK_Y0 = YF + WALL
px0, px1 = BX0 + WALL, BX1 - 6.5
col_w = (px1 - px0 - 3 * RIB) / 4.0
z_lo = Z_SLOPE + 1.0
for i in range(4):
    x0 = px0 + i * (col_w + RIB)
    # lowest (tall) pocket follows the sloped front
    cutters.append(prism_yz([(POCK_Y0, 93.5), (YB + 1, 93.5), (YB + 1, 56.0),
                             (y_slope(56.0) + 3.5, 56.0), (POCK_Y0, z_lo)],
                            x0, x0 + col_w))
    upper = [(112.5, 159.0)] if i in (1, 2) else [(112.5, 136.0), (138.5, 159.0)]
    for (z0, z1) in [(96.0, 110.0)] + upper:
        cutters.append(box(x0, x0 + col_w, POCK_Y0, YB + 1, z0, z1))
# top window between the two walls (inner ribs are kept lower there)
cutters.append(box(22.35, 53.85, YF - 1, 5.0, 148.7, 185.0))
cutters.append(box(22.35, 53.85, POCK_Y0, YB + 1, 129.0, 160.0))
# cable notch on the +X side
NOTCH_Z, NOTCH_D, NOTCH_R, NOTCH_F = 123.15, 10.0, 8.0, 5.0
_F = (YB - NOTCH_F, 0.0)
_N = (YB - NOTCH_D + NOTCH_R, 0.0)
_dz = math.sqrt((NOTCH_R + NOTCH_F) ** 2 - (NOTCH_D - NOTCH_F - NOTCH_R) ** 2)
_u = ((_N[0] - _F[0]) / (NOTCH_R + NOTCH_F), -_dz / (NOTCH_R + NOTCH_F))
_Tu = (_F[0] + NOTCH_F * _u[0], NOTCH_Z + _dz + NOTCH_F * _u[1])
_Td = (_Tu[0], 2 * NOTCH_Z - _Tu[1])
_a = math.atan2(_u[1], _u[0]) / 2.0
_Mu = (_F[0] + NOTCH_F * math.cos(_a), NOTCH_Z + _dz + NOTCH_F * math.sin(_a))
_Md = (_Mu[0], 2 * NOTCH_Z - _Mu[1])
cutters.append(cq.Workplane("YZ", origin=(BX0, 0, 0))
               .moveTo(YB + 2.0, NOTCH_Z + _dz).lineTo(YB, NOTCH_Z + _dz)
               .threePointArc(_Mu, _Tu)
               .threePointArc((YB - NOTCH_D, NOTCH_Z), _Td)
               .threePointArc(_Md, (YB, NOTCH_Z - _dz))
               .lineTo(YB + 2.0, NOTCH_Z - _dz).close()
               .extrude(BX1 - BX0 + 1.0))
# two big holes through the lower section (horizontal, along Y)
for hx in BIG_HOLE_X:
    cutters.append(cyl_solid((hx, YF - 5, BIG_HOLE_Z), (0, 1, 0), BIG_HOLE_D, 60))
# two holes in the arm, square to its top face
n_arm = cq.Vector(0, ARM_K, 1).normalized()
for hx in (-38.15, -22.55):
    ytop = -14.7
    p = cq.Vector(hx, ytop, arm_z(ytop, ARM_ZT)) + n_arm * 3
    cutters.append(cyl_solid(p.toTuple(), (-n_arm).toTuple(), 5.5, 22))
# triangular truss opening in the rear part of the arm
cutters.append(prism_xy([(-40.0, -4.8), (-10.6, -4.8), (-10.6, 14.3)], 70, 115))
block = block.cut(group(cutters))

# concave fillet where the lower wedge meets the back of the front block
FIL_R = 6.0
fil = box(BX0, BX1, YB - 0.2, YB + FIL_R, Z_WEDGE_TOP - 0.2, Z_WEDGE_TOP + FIL_R)
fil = fil.cut(group([cyl_solid((BX0 - 1, YB + FIL_R, Z_WEDGE_TOP + FIL_R),
                               (1, 0, 0), 2 * FIL_R, BX1 - BX0 + 2)]))
# thin cross ribs (parallel to the front) in the cells under the top window
x_r0 = px0 + (col_w + RIB) - 0.2
x_r1 = px0 + 3 * col_w + 2 * RIB + 0.2
block = block.union(group([fil] + [box(x_r0, x_r1, yr - 0.6, yr + 0.6, 111.0, 129.0)
                                   for yr in (-19.8, -14.1)]))

# rounded inner top edges of the two walls beside the top window
for wx in (22.35, 53.85):
    block = block.edges(cq.selectors.BoxSelector((wx - 0.3, -24.0, 162.0),
                                                 (wx + 0.3, -6.0, 169.5))).fillet(4.0)

# engraved version mark on the +X side
try:
    txt = (cq.Workplane(cq.Plane(origin=(BX1, -18.0, 95.5), xDir=(0, 0, -1),
                                 normal=(1, 0, 0)))
           .text("V1.1", 12.7, -0.8, font="DejaVu Sans", combine=False,
                 halign="center", valign="center"))
    block = block.cut(txt)
except Exception:
    pass

# ---------------------------------------------------------------------------
# Top frame: wedge box made of a tilted front X-plate and a vertical back plate
# ---------------------------------------------------------------------------
fr_prof = [(3.0, Z_BLK_TOP), (FR_YB, Z_BLK_TOP), (FR_YB, H_TOP),
           (frame_y(H_TOP), H_TOP), (frame_y(FR_ZC), FR_ZC)]
frame = prism_yz(fr_prof, XL, XR)
y_in0 = FR_Y0 + FR_T / 0.9777
z_meet = Z_BLK_TOP + ((FR_YB - FR_T) - y_in0) / FR_K
FR_FLOOR = 172.0                               # trough floor inside the frame
fr_cut = [prism_yz([(y_in0 + (FR_FLOOR - Z_BLK_TOP) * FR_K, FR_FLOOR),
                    (FR_YB - FR_T, FR_FLOOR - 6.0),
                    (FR_YB - FR_T, z_meet)], XL + FR_T, XR - FR_T)]
# X-brace openings of the tilted front plate (cut only through that plate)
openings = [
    [(-47.75, 226.7), (47.85, 226.7), (25.65, 216.0), (-25.55, 216.0)],
    [(-58.35, 217.4), (-56.75, 181.1), (-11.35, 199.1)],
    [(58.35, 217.4), (56.75, 181.1), (11.35, 199.1)],
    [(-46.75, 172.2), (46.75, 172.2), (0.0, 194.4)],
]
front_slab = prism_yz([(frame_y(160.0) - 1.5, 160.0), (frame_y(H_TOP + 2) - 1.5, H_TOP + 2),
                       (frame_y(H_TOP + 2) + FR_T / 0.9777 + 0.4, H_TOP + 2),
                       (frame_y(160.0) + FR_T / 0.9777 + 0.4, 160.0)], XL - 1, XR + 1)
for op in openings:
    fr_cut.append(prism_xz(op, -12.0, FR_YB + 2.0).intersect(front_slab))
# corner-to-corner X brace of the vertical back plate
BK_BX, BK_Z0, BK_Z1 = 58.0, 170.3, 229.5        # back bolt pattern
back_openings = [
    [(-49.0, 231.0), (49.0, 231.0), (0.0, 202.7)],
    [(-47.0, 170.0), (47.0, 170.0), (0.0, 197.1)],
    [(-63.0, 221.0), (-63.0, 179.0), (-8.0, 199.9)],
    [(63.0, 221.0), (63.0, 179.0), (8.0, 199.9)],
]
behind_front = prism_yz([(frame_y(160.0) + FR_T / 0.9777 + 0.3, 160.0),
                         (frame_y(H_TOP + 2) + FR_T / 0.9777 + 0.3, H_TOP + 2),
                         (FR_YB + 2.0, H_TOP + 2), (FR_YB + 2.0, 160.0)], XL - 1, XR + 1)
for op in back_openings:
    fr_cut.append(prism_xz(op, FR_YB - FR_T - 0.6, FR_YB + 1.0).intersect(behind_front))
frame = frame.cut(group(fr_cut))

# ---------------------------------------------------------------------------
# Brackets under the back of the frame
# ---------------------------------------------------------------------------
bbr = prism_yz([(7.6, Z_BLK_TOP + 0.5), (28.8, Z_BLK_TOP + 0.5), (28.8, 149.1),
                (7.6, Z_BLK_TOP - 0.2)], XL, -5.85)
bbr = bbr.cut(group([
    prism_xy([(-62.4, 29.5), (-70.5, 29.5), (-70.5, 17.4)], 140, 170),
    cyl_solid((-49.9, 22.7, 140), (0, 0, 1), 5.5, 30)]))

# ---------------------------------------------------------------------------
# Bolts
# ---------------------------------------------------------------------------
n_front = (0.0, -0.9777, 0.2102)
n_slope = (0.0, -1.0 / math.sqrt(1 + K_SLOPE ** 2),
           -K_SLOPE / math.sqrt(1 + K_SLOPE ** 2))
bolts = []
for bx in (-59.5, 59.5):
    for bz in (224.5, 179.5):
        bolts += bolt_solids((bx, frame_y(bz), bz), n_front)
for bx in (-BK_BX, BK_BX):
    for bz in (BK_Z1, BK_Z0):
        bolts += bolt_solids((bx, FR_YB, bz), (0, 1, 0), head_d=11.0)
for bx in (16.9, 56.5):
    for bz in (153.6, 80.75):
        bolts += bolt_solids((bx, YF, bz), (0, -1, 0))
for bx in (3.45, 56.75):
    for bz in (51.6, 7.0):
        bolts += bolt_solids((bx, y_slope(bz), bz), n_slope)
bolts.append(cyl_solid((-34.9, 28.0, 156.5), (0, 1, 0), 5.0, 6.1))

result = block.union(group([frame, bbr] + bolts))

VIEW = {"azimuth": 45, "elevation": 26}
